import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 237.0          # front plate width  (X)
H = 128.0          # front plate height (Z)
T1 = 3.8           # front plate thickness
GAP = 5.9          # gap between front and back plate
T2 = 3.8           # back plate thickness

R_CORNER = 13.6    # concave corner relief radius (centred on plate corner)
R_NOTCH = 10.6     # concave centre notch radius (top & bottom edge)
X_NOTCH = -2.1     # centre notch X position
R_OUT_FIL = 2.9    # fillet on the convex points of the outline

D_HOLE = 3.2       # small mounting holes
HOLE_Z = 57.1
HOLE_X = [-102.0, -19.85, 15.7, 99.0]

# window (in the -X half)
WIN_X0, WIN_X1 = -92.3, 0.3
WIN_H = 64.6
WIN_R = 2.3
FL_T = 1.5         # window flange sheet thickness
FL_FRONT = 1.9     # flange protrusion in front of the front face
FL_TB_X0, FL_TB_X1 = -78.5, -13.1   # top/bottom flange extent
FL_LR_H = 49.3                      # left/right flange height

# stand-off bosses
BOSS_X = [-99.2, 6.9]
BOSS_Z = 36.9
BOSS_D = 10.4
BOSS_L = 13.1      # protrusion in front of the front face
BOSS_FIL = 1.5
BOSS_HOLE = 4.0

# back plate (two stepped rectangles)
BP_X0, BP_XS, BP_X1 = -108.0, 16.0, 87.5
BP_H_WIN = 96.2    # height of window pad part
BP_H_RIGHT = 59.0  # height of +X part
BP_R = 3.0

# posts between plates in +X half
POST_X = [36.5, 77.5]
POST_T = 2.2
POST_H = 41.3

# clip (hat channel) on the +X half
CLIP_XC = 57.25
CLIP_H = 41.3
CLIP_WALL = 8.1    # half width to wall outer face
CLIP_D = 6.9       # protrusion
CLIP_T = 1.8
CLIP_R_IN = 0.3    # inner bend radius
CLIP_R_OUT = 1.6   # outer bend radius
CLIP_R_ROOT = 1.2  # root bend radius into the plate

Y_BP0 = T1 + GAP          # back plate front face
Y_BP1 = T1 + GAP + T2     # back plate back face


def xz_wp(y):
    """workplane parallel to XZ whose extrude goes toward +Y when distance<0"""
    return cq.Workplane("XZ", origin=(0, y, 0))


# ---------------- front plate ----------------
outline = (
    cq.Sketch()
    .rect(W, H)
    .push([(W / 2, H / 2), (-W / 2, H / 2), (W / 2, -H / 2), (-W / 2, -H / 2)])
    .circle(R_CORNER, mode="s")
    .push([(X_NOTCH, H / 2), (X_NOTCH, -H / 2)])
    .circle(R_NOTCH, mode="s")
    .reset()
    .vertices()
    .fillet(R_OUT_FIL)
)
front = xz_wp(T1).placeSketch(outline).extrude(T1)   # Y from 0 .. T1

# ---------------- bosses ----------------
for bx in BOSS_X:
    for bz in (BOSS_Z, -BOSS_Z):
        cyl = (
            cq.Workplane("XZ", origin=(bx, 0, bz))
            .circle(BOSS_D / 2)
            .extrude(BOSS_L)
        )
        front = front.union(cyl)

# fillet boss roots on the front face
front = front.edges(
    cq.selectors.BoxSelector((-W, -0.01, -H), (W, 0.01, H))
).edges("%CIRCLE").fillet(BOSS_FIL)

# stand-off part of the bosses in the gap
for bx in BOSS_X:
    for bz in (BOSS_Z, -BOSS_Z):
        cyl = (
            cq.Workplane("XZ", origin=(bx, Y_BP0 + 0.01, bz))
            .circle(BOSS_D / 2)
            .extrude(GAP + 0.02)
        )
        front = front.union(cyl)

# ---------------- small holes ----------------
pts = [(x, z) for x in HOLE_X for z in (HOLE_Z, -HOLE_Z)]
holes = xz_wp(T1 + 1).pushPoints(pts).circle(D_HOLE / 2).extrude(T1 + 2)
front = front.cut(holes)

# ---------------- window ----------------
WIN_XC = (WIN_X0 + WIN_X1) / 2
WIN_W = WIN_X1 - WIN_X0
win_cut = (
    xz_wp(Y_BP1 + 1)
    .center(WIN_XC, 0)
    .sketch()
    .rect(WIN_W, WIN_H)
    .vertices()
    .fillet(WIN_R)
    .finalize()
    .extrude(Y_BP1 + 2)
)

# ---------------- back plate ----------------
hw, hr = BP_H_WIN / 2, BP_H_RIGHT / 2
bp_pts = [
    (BP_X0, -hw), (BP_XS, -hw), (BP_XS, -hr), (BP_X1, -hr),
    (BP_X1, hr), (BP_XS, hr), (BP_XS, hw), (BP_X0, hw),
]
back = xz_wp(Y_BP1).polyline(bp_pts).close().extrude(T2)
back = back.edges("|Y").fillet(BP_R)

body = front.union(back).cut(win_cut)

# ---------------- window flanges ----------------
fl_len_y = Y_BP1 + FL_FRONT
fl_y0 = -FL_FRONT
tb_len = FL_TB_X1 - FL_TB_X0
for zs in (1, -1):
    zc = zs * (WIN_H / 2 - FL_T / 2)
    b = cq.Workplane("XY").box(tb_len, fl_len_y, FL_T).translate(
        ((FL_TB_X0 + FL_TB_X1) / 2, fl_y0 + fl_len_y / 2, zc)
    )
    body = body.union(b)
for xc in (WIN_X0 + FL_T / 2, WIN_X1 - FL_T / 2):
    b = cq.Workplane("XY").box(FL_T, fl_len_y, FL_LR_H).translate(
        (xc, fl_y0 + fl_len_y / 2, 0)
    )
    body = body.union(b)

# ---------------- posts in +X half ----------------
for px in POST_X:
    b = cq.Workplane("XY").box(POST_T, GAP + 0.2, POST_H).translate(
        (px, T1 + GAP / 2, 0)
    )
    body = body.union(b)

# ---------------- clip (formed U-bridge) ----------------
a = CLIP_WALL
t = CLIP_T
d = CLIP_D
prof = [
    (-a, 0.5), (-a, -d), (a, -d), (a, 0.5),
    (a - t, 0.5), (a - t, -d + t), (-a + t, -d + t), (-a + t, 0.5),
]
clip = (
    cq.Workplane("XY", origin=(CLIP_XC, 0, -CLIP_H / 2))
    .polyline(prof)
    .close()
    .extrude(CLIP_H)
)
# outer bends
clip = clip.edges(cq.selectors.BoxSelector(
    (CLIP_XC - a - 0.01, -d - 0.01, -CLIP_H), (CLIP_XC + a + 0.01, -d + 0.01, CLIP_H)
)).edges("|Z").fillet(CLIP_R_OUT)
# inner bends
clip = clip.edges(cq.selectors.BoxSelector(
    (CLIP_XC - a + t - 0.01, -d + t - 0.01, -CLIP_H), (CLIP_XC + a - t + 0.01, -d + t + 0.01, CLIP_H)
)).edges("|Z").fillet(CLIP_R_IN)
body = body.union(clip)
# root bends blending the bridge legs into the plate
body = body.edges(cq.selectors.BoxSelector(
    (CLIP_XC - a - 0.01, -0.01, -CLIP_H), (CLIP_XC - a + 0.01, 0.01, CLIP_H)
)).fillet(CLIP_R_ROOT)
body = body.edges(cq.selectors.BoxSelector(
    (CLIP_XC + a - 0.01, -0.01, -CLIP_H), (CLIP_XC + a + 0.01, 0.01, CLIP_H)
)).fillet(CLIP_R_ROOT)

# ---------------- boss holes ----------------
for bx in BOSS_X:
    for bz in (BOSS_Z, -BOSS_Z):
        hole = (
            cq.Workplane("XZ", origin=(bx, Y_BP0, bz))
            .circle(BOSS_HOLE / 2)
            .extrude(Y_BP0 + BOSS_L + 1)
        )
        body = body.cut(hole)

result = body
